import cadquery as cq

# Stepped square wall cover plate (86-type), standing upright in the XZ plane.
# Back face is flat at Y = 0, the three stepped frames rise toward -Y (front),
# with a square pocket in the front and two small through openings.

# ---------------- driving dimensions (mm) ----------------
W1 = 86.0        # back plate (largest step) square size
W2 = 78.6        # middle step size
W3 = 71.0        # front step size
T_STEP = 3.0     # thickness of each step
R_CORNER = 2.4   # plan-view corner radius of every step
R_FRONT = 2.1    # round on the front edge of each step
R_BACK = 0.3     # small round on the back edge of each step

POCKET = 63.4        # square pocket in the front face (sharp corners)
POCKET_DEPTH = 5.9   # measured from the front face

SQ_HOLE = 3.5                # small square through hole
SQ_X, SQ_Z = 1.65, 3.4       # its centre (right of and above plate centre)
SLOT_W, SLOT_H = 7.4, 3.3    # rectangular through slot
SLOT_X, SLOT_Z = 0.0, -3.0   # its centre (below plate centre)

# recesses in the back face around the openings
BREC_W, BREC_H = 6.8, 3.6    # rectangular recess around the square hole
BREC_X, BREC_Z = 0.1, SQ_Z
OVAL_W, OVAL_H = 9.9, 7.6    # oval recess around the slot
BACK_REC_DEPTH = 1.5

THROUGH = 30.0   # generous length for through cuts


def slab(size, y_back, t):
    """Rounded-corner square slab, back face at y_back, extending toward -Y."""
    s = (cq.Workplane("XZ", origin=(0, y_back, 0))   # XZ normal is -Y
         .rect(size, size).extrude(t)
         .edges("|Y").fillet(R_CORNER))
    s = s.faces("<Y").edges().fillet(R_FRONT)       # front edge round
    s = s.faces(">Y").edges().fillet(R_BACK)        # back edge break
    return s


# ---------------- stepped body ----------------
body = slab(W1, 0.0, T_STEP)
body = body.union(slab(W2, -T_STEP, T_STEP))
body = body.union(slab(W3, -2 * T_STEP, T_STEP))
y_front = -3 * T_STEP

# ---------------- front pocket ----------------
pocket = (cq.Workplane("XZ", origin=(0, y_front + POCKET_DEPTH, 0))
          .rect(POCKET, POCKET).extrude(POCKET_DEPTH + 1.0))
body = body.cut(pocket)

# ---------------- through openings ----------------
cut_wp = cq.Workplane("XZ", origin=(0, THROUGH / 2, 0))
sq = cut_wp.center(SQ_X, SQ_Z).rect(SQ_HOLE, SQ_HOLE).extrude(THROUGH)
slot = cut_wp.center(SLOT_X, SLOT_Z).rect(SLOT_W, SLOT_H).extrude(THROUGH)
body = body.cut(sq).cut(slot)

# ---------------- back-face recesses ----------------
back_wp = cq.Workplane("XZ", origin=(0, 1.0, 0))   # start just behind the back face
brec = (back_wp.center(BREC_X, BREC_Z).rect(BREC_W, BREC_H)
        .extrude(1.0 + BACK_REC_DEPTH))
oval = (back_wp.center(SLOT_X, SLOT_Z).ellipse(OVAL_W / 2, OVAL_H / 2)
        .extrude(1.0 + BACK_REC_DEPTH))
body = body.cut(brec).cut(oval)

result = body
